import math
import cadquery as cq
from OCP.BRep import BRep_Tool
from OCP.BRepAdaptor import BRepAdaptor_Curve
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.Geom import Geom_TrimmedCurve
from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
from OCP.BRepPrimAPI import BRepPrimAPI_MakeCone, BRepPrimAPI_MakeCylinder
from OCP.gp import gp_Ax2, gp_Pnt, gp_Dir

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # plate width (X)
H = 100.0          # plate height (Z)
T = 13.3           # plate thickness (Y); front face at -Y, back face at +Y
R_CORNER = 12.0    # corner radius of the square outline

# corner mounting holes (through, along Y)
CH_OFF = 36.6      # offset of the hole centres from the plate centre
CH_D = 8.4

# two small blind holes in the centre of the front face
FH_PITCH = 10.0
FH_D = 6.3
FH_DEPTH = 6.0

# rectangular pocket in the back face
PK_W = 33.4
PK_H = 16.9
PK_DEPTH = 3.1

# edge ports (two on every edge face), slightly behind the mid-plane
EP_OFF = 11.7      # offset of each port from the centre line
EP_Y = 0.85        # port axis offset toward the back face
EP_D = 7.05        # port bore
EP_DEPTH = 7.0     # flat-bottom depth of the side ports
EP_PILOT_D = 2.4   # small pilot of the side ports
EP_PILOT_LEN = 10.0
EP_STEP_D = 4.1    # extra step in the lower side ports
EP_STEP_LEN = 1.5
TB_CONE_HALF = 17.0  # top / bottom ports: steep tapered (conical) seat
DRILL_ANGLE = 118.0

# engraved roman numerals on the front face
TXT_H = 3.5
TXT_STEM = 0.5
TXT_SERIF_W = 1.35
TXT_SERIF_H = 0.45
TXT_DEPTH = 0.3
TXT_I_X = 37.5      # centre of "I"
TXT_II_X = -36.3    # centre of "II"
TXT_II_PITCH = 1.5
TXT_Z = -1.0

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- outline: rounded square as one smooth closed curve --------
def rounded_square_edge(w, h, r):
    """Lines + tangent arcs joined into a single exact (rational) B-spline
    edge, so the side wall is one smooth face."""
    hw, hh = w / 2.0, h / 2.0
    V = cq.Vector
    c = r * math.cos(math.pi / 4.0)
    # start / end (the seam of the side wall) at the middle of the lower-left
    # corner arc, where it is least exposed
    q = math.sin(math.pi / 8.0) * r
    k = math.cos(math.pi / 8.0) * r
    m0 = V(-hw + r - c, 0, -hh + r - c)
    segs = [
        cq.Edge.makeThreePointArc(m0, V(-hw + r - q, 0, -hh + r - k), V(-hw + r, 0, -hh)),
        cq.Edge.makeLine(V(-hw + r, 0, -hh), V(hw - r, 0, -hh)),
        cq.Edge.makeThreePointArc(V(hw - r, 0, -hh), V(hw - r + c, 0, -hh + r - c), V(hw, 0, -hh + r)),
        cq.Edge.makeLine(V(hw, 0, -hh + r), V(hw, 0, hh - r)),
        cq.Edge.makeThreePointArc(V(hw, 0, hh - r), V(hw - r + c, 0, hh - r + c), V(hw - r, 0, hh)),
        cq.Edge.makeLine(V(hw - r, 0, hh), V(-hw + r, 0, hh)),
        cq.Edge.makeThreePointArc(V(-hw + r, 0, hh), V(-hw + r - c, 0, hh - r + c), V(-hw, 0, hh - r)),
        cq.Edge.makeLine(V(-hw, 0, hh - r), V(-hw, 0, -hh + r)),
        cq.Edge.makeThreePointArc(V(-hw, 0, -hh + r), V(-hw + r - k, 0, -hh + r - q), m0),
    ]
    conv = None
    for seg in segs:
        crv = BRep_Tool.Curve_s(seg.wrapped, 0.0, 0.0)
        ad = BRepAdaptor_Curve(seg.wrapped)
        tc = Geom_TrimmedCurve(crv, ad.FirstParameter(), ad.LastParameter())
        if conv is None:
            conv = GeomConvert_CompCurveToBSplineCurve(tc)
        else:
            conv.Add(tc, 1e-7, True)
    return cq.Edge(BRepBuilderAPI_MakeEdge(conv.BSplineCurve()).Edge())


outline = cq.Wire.assembleEdges([rounded_square_edge(W, H, R_CORNER)])
base_face = cq.Face.makeFromWires(outline).translate(cq.Vector(0, -T / 2.0, 0))
plate = cq.Workplane("XY").add(cq.Solid.extrudeLinear(base_face, cq.Vector(0, T, 0)))

# ---------------- corner through holes ----------------
corner_pts = [(sx * CH_OFF, sz * CH_OFF) for sx in (-1, 1) for sz in (-1, 1)]
holes = (
    cq.Workplane("XZ")
    .pushPoints(corner_pts)
    .circle(CH_D / 2.0)
    .extrude(T, both=True)
)
plate = plate.cut(holes)

# ---------------- front face (-Y) blind holes ----------------
front_wp = cq.Workplane("XZ", origin=(0, -T / 2.0, 0))
fh = (
    front_wp.pushPoints([(-FH_PITCH / 2.0, 0), (FH_PITCH / 2.0, 0)])
    .circle(FH_D / 2.0)
    .extrude(-FH_DEPTH)
)
plate = plate.cut(fh)

# ---------------- back face (+Y) rectangular pocket ----------------
back_wp = cq.Workplane("XZ", origin=(0, T / 2.0, 0))
pk = back_wp.rect(PK_W, PK_H).extrude(PK_DEPTH)
plate = plate.cut(pk)


# ---------------- edge ports ----------------
def _ax(o, n, xdir):
    return gp_Ax2(gp_Pnt(o.x, o.y, o.z), gp_Dir(n.x, n.y, n.z), gp_Dir(xdir.x, xdir.y, xdir.z))


def cyl(r, h, o, n, xdir):
    """Cylinder whose seam lies along xdir (kept out of sight)."""
    return cq.Solid(BRepPrimAPI_MakeCylinder(_ax(o, n, xdir), r, h).Shape())


def cone(r1, r2, h, o, n, xdir):
    return cq.Solid(BRepPrimAPI_MakeCone(_ax(o, n, xdir), r1, r2, h).Shape())


def tapered_port(origin, direction, xdir):
    """Port with a steep conical (tapered) seat starting at the face."""
    o = cq.Vector(*origin)
    n = cq.Vector(*direction).normalized()
    xd = cq.Vector(*xdir).normalized()
    cone_h = (EP_D / 2.0) / math.tan(math.radians(TB_CONE_HALF))
    return cone(EP_D / 2.0, 0.0, cone_h, o, n, xd)


def side_port(origin, direction, xdir, stepped):
    """Flat-bottom counterbored port with a small pilot; the lower ports
    have an extra step and a conical transition."""
    o = cq.Vector(*origin)
    n = cq.Vector(*direction).normalized()
    xd = cq.Vector(*xdir).normalized()
    s = cyl(EP_D / 2.0, EP_DEPTH, o, n, xd)
    start = EP_DEPTH
    if stepped:
        s = s.fuse(cyl(EP_STEP_D / 2.0, EP_STEP_LEN, o + n * start, n, xd))
        start += EP_STEP_LEN
        cone_h = (EP_STEP_D - EP_PILOT_D) / 2.0 / math.tan(math.radians(DRILL_ANGLE / 2.0))
        s = s.fuse(cone(EP_STEP_D / 2.0, EP_PILOT_D / 2.0, cone_h, o + n * start, n, xd))
    s = s.fuse(cyl(EP_PILOT_D / 2.0, EP_PILOT_LEN, o + n * start, n, xd))
    return s


ports = []
for sx in (-1, 1):
    # top and bottom faces
    ports.append(tapered_port((sx * EP_OFF, EP_Y, H / 2.0), (0, 0, -1), (1, 1, 0)))
    ports.append(tapered_port((sx * EP_OFF, EP_Y, -H / 2.0), (0, 0, 1), (1, 1, 0)))
for sx in (-1, 1):
    # right (+X) and left (-X) faces
    ports.append(side_port((sx * W / 2.0, EP_Y, EP_OFF), (-sx, 0, 0), (0, -sx, 0), False))
    ports.append(side_port((sx * W / 2.0, EP_Y, -EP_OFF), (-sx, 0, 0), (0, -sx, 0), True))
for p in ports:
    plate = plate.cut(cq.Workplane("XY").add(p))


# ---------------- engraved roman numerals ----------------
def roman_one(cx, cz):
    wp = cq.Workplane("XZ", origin=(0, -T / 2.0, 0))
    stem = wp.center(cx, cz).rect(TXT_STEM, TXT_H).extrude(-TXT_DEPTH)
    dz = (TXT_H - TXT_SERIF_H) / 2.0
    top = wp.center(cx, cz + dz).rect(TXT_SERIF_W, TXT_SERIF_H).extrude(-TXT_DEPTH)
    bot = wp.center(cx, cz - dz).rect(TXT_SERIF_W, TXT_SERIF_H).extrude(-TXT_DEPTH)
    return stem.union(top).union(bot)


txt = roman_one(TXT_I_X, TXT_Z)                                   # "I"
txt = txt.union(roman_one(TXT_II_X - TXT_II_PITCH / 2.0, TXT_Z))  # "II"
txt = txt.union(roman_one(TXT_II_X + TXT_II_PITCH / 2.0, TXT_Z))
plate = plate.cut(txt)

result = plate
